import math
import cadquery as cq

# ---- driving dimensions (mm) ----
D = 60.0            # outer (tip) diameter of the knurled knob
H = 15.8            # overall height
N = 60              # number of flutes
GROOVE_R = 1.17     # radius of each flute (concave cylindrical groove)
GROOVE_OFF = 0.0    # groove centre lies this far outside the tip circle

REC1_D = 38.2       # underside counterbore diameter
REC1_DEPTH = 8.0    # underside counterbore depth
REC2_D = 32.1       # inner (deeper) bore diameter
REC2_DEPTH = 9.55   # total depth of the inner bore from the underside

R = D / 2.0
rc = R + GROOVE_OFF          # radius of the groove-centre circle
pitch = 2 * math.pi / N

# half-angle at which a groove circle meets the tip circle
half = math.acos((R * R + rc * rc - GROOVE_R * GROOVE_R) / (2 * R * rc))


def pol(r, a):
    return (r * math.cos(a), r * math.sin(a))


# fluted outline: alternating land arcs (tip circle) and concave groove arcs
wp = cq.Workplane("XY").moveTo(*pol(R, half))
for i in range(N):
    a0 = i * pitch
    la, lb = a0 + half, a0 + pitch - half
    wp = wp.threePointArc(pol(R, 0.5 * (la + lb)), pol(R, lb))
    ga = a0 + pitch
    wp = wp.threePointArc(pol(rc - GROOVE_R, ga), pol(R, ga + half))
body = wp.close().extrude(H)

# ---- underside recess (stepped) ----
rec1 = cq.Workplane("XY").circle(REC1_D / 2.0).extrude(REC1_DEPTH)
rec2 = cq.Workplane("XY").circle(REC2_D / 2.0).extrude(REC2_DEPTH)
body = body.cut(rec1).cut(rec2)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
